import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Gear-sector lever (sector gear with bent arm)
# Origin = gear / pivot centre, plate lies in XY, thickness along +Z
# ---------------------------------------------------------------------------

T = 20.0                 # plate thickness

# gear sector
N_TEETH_FULL = 48        # teeth on the full circle
PITCH = 360.0 / N_TEETH_FULL
MODULE = 1.25
R_PITCH = MODULE * N_TEETH_FULL / 2.0   # 30
R_TIP = R_PITCH + MODULE                # 31.25
R_ROOT = 28.4                           # 1.25 m dedendum
N_SECTOR = 18            # teeth actually cut on the sector
FIRST_TOOTH_ANG = 89.5   # angle of the first tooth (next to the prong)
SECTOR_END_ANG = 220.5   # root arc ends here (start of the lower flank line)

# pivot bore: through hole with counterbore on both faces
BORE_D = 7.0
CBORE_D = 17.5
CBORE_DEPTH = 5.6
DRILL_POINT = 118.0      # included angle of the drilled bottom counterbore

# fixing holes along the arm
HOLE_D = 7.0
HOLES = [(20.45, -23.05), (34.3, -81.35), (32.65, -101.55)]

# outline corner points (mm)
P_PRONG_L = (2.6, 42.5)      # prong tip, left corner
P_PRONG_R = (5.9, 43.85)     # prong tip, right corner
P_BEND_R1 = (36.4, -19.85)   # right edge first (sharp) bend
P_BEND_R2 = (45.1, -67.6)    # right edge second (rounded) bend
P_TAIL_R = (40.75, -127.5)   # tail, outer corner
P_TAIL_L = (20.5, -106.4)    # tail, inner corner
P_BEND_L = (23.45, -64.6)    # left edge bend
P_NOTCH = (7.3, -20.95)      # inside corner under the gear sector

R_BEND_R = 35.0
R_BEND_L = 32.0
R_TAIL_R = 4.7
R_TAIL_L = 6.0
R_NOTCH = 6.0
R_PRONG_ROOT = 1.5


def prong_root_point():
    """Point where the prong's left edge meets the root circle."""
    x0, y0 = P_PRONG_L
    # prong left edge direction (going down)
    dx, dy = 0.127, -1.0
    n = math.hypot(dx, dy)
    dx, dy = dx / n, dy / n
    # solve |p0 + t d| = R_ROOT
    b = 2 * (x0 * dx + y0 * dy)
    c = x0 * x0 + y0 * y0 - R_ROOT ** 2
    t = (-b - math.sqrt(b * b - 4 * c)) / 2
    return (x0 + t * dx, y0 + t * dy)


def polar(r, a):
    return (r * math.cos(math.radians(a)), r * math.sin(math.radians(a)))


P_PRONG_ROOT = prong_root_point()
a_start = math.degrees(math.atan2(P_PRONG_ROOT[1], P_PRONG_ROOT[0]))
P_SECTOR_END = polar(R_ROOT, SECTOR_END_ANG)
P_ARC_MID = polar(R_ROOT, 0.5 * (a_start + SECTOR_END_ANG))

# ---------------------------------------------------------------- main plate
body = (
    cq.Workplane("XY")
    .moveTo(*P_TAIL_R)
    .lineTo(*P_BEND_R2)
    .lineTo(*P_BEND_R1)
    .lineTo(*P_PRONG_R)
    .lineTo(*P_PRONG_L)
    .lineTo(*P_PRONG_ROOT)
    .threePointArc(P_ARC_MID, P_SECTOR_END)
    .lineTo(*P_NOTCH)
    .lineTo(*P_BEND_L)
    .lineTo(*P_TAIL_L)
    .close()
    .extrude(T)
)


def fillet_at(wp, pt, r):
    return (
        wp.edges("|Z")
        .edges(cq.selectors.NearestToPointSelector((pt[0], pt[1], T / 2)))
        .fillet(r)
    )


body = fillet_at(body, P_BEND_R2, R_BEND_R)
body = fillet_at(body, P_BEND_L, R_BEND_L)
body = fillet_at(body, P_TAIL_R, R_TAIL_R)
body = fillet_at(body, P_TAIL_L, R_TAIL_L)
body = fillet_at(body, P_NOTCH, R_NOTCH)
body = fillet_at(body, P_PRONG_L, 0.6)
body = fillet_at(body, P_PRONG_ROOT, R_PRONG_ROOT)

# ---------------------------------------------------------------- gear teeth
def tooth(angle):
    """One tooth, axis along +X, then rotated to `angle`."""
    r0 = R_ROOT - 0.4
    w_root = 1.40      # half widths (mm)
    w_pitch = 0.98
    w_tip = 0.72
    rt = R_TIP - 0.38
    prof = (
        cq.Workplane("XY")
        .moveTo(r0, -w_root)
        .threePointArc((R_PITCH, -w_pitch), (rt, -w_tip))
        .threePointArc((R_TIP, 0.0), (rt, w_tip))
        .threePointArc((R_PITCH, w_pitch), (r0, w_root))
        .close()
        .extrude(T)
    )
    return prof.rotate((0, 0, 0), (0, 0, 1), angle)


for k in range(N_SECTOR):
    body = body.union(tooth(FIRST_TOOTH_ANG + k * PITCH))

# ---------------------------------------------------------------- holes
# pivot bore: flat counterbore from the top face, drilled counterbore
# (118 deg drill point) from the bottom face, 7 mm through bore between
_h_cone = (CBORE_D - BORE_D) / 2 / math.tan(math.radians(DRILL_POINT / 2))
bore_profile = (
    cq.Workplane("XZ")
    .polyline([
        (0, -1.0),
        (CBORE_D / 2, -1.0),
        (CBORE_D / 2, CBORE_DEPTH),
        (BORE_D / 2, CBORE_DEPTH + _h_cone),
        (BORE_D / 2, T - CBORE_DEPTH),
        (CBORE_D / 2, T - CBORE_DEPTH),
        (CBORE_D / 2, T + 1.0),
        (0, T + 1.0),
    ])
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)
body = body.cut(bore_profile)

for (hx, hy) in HOLES:
    body = body.cut(
        cq.Workplane("XY").center(hx, hy).circle(HOLE_D / 2).extrude(T)
    )

result = body

VIEW = {"azimuth": 45, "elevation": 26}
